import cadquery as cq

# =====================================================================
#  Flat mounting plate with centre notches top/bottom, two side notches
#  on each long edge (the tab between them bevelled on the back), a
#  pattern of small through holes and four rounded-square windows.
#  The plate stands upright in the XZ plane, thickness along Y.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 158.6          # plate width  (X)
H = 220.0          # plate height (Z)
T = 6.3            # plate thickness (Y)
R_CORNER = 11.0    # outer corner radius

# top / bottom centre notches
TN_W = 44.0        # notch width
TN_D = 19.5        # notch depth
TN_R_OUT = 4.2     # fillet where notch meets the top/bottom edge
TN_R_IN = 3.7      # fillet at notch bottom corners

# side notches (two on each long edge, symmetric about Z=0)
SN_Z = 22.1        # notch centre height (+/-)
SN_W = 17.2        # notch width (along Z)
SN_D = 6.0         # notch depth (along X)
SN_R = 2.0         # fillets on the side notches

# bevel on the back edge of the tab left between the two side notches
BV_X = 5.2         # bevel width measured on the back face (X)
BV_Y = 2.6         # bevel height measured on the edge face (Y)

# holes
HOLE_D = 4.0       # small round through holes
E_CORNER = 9.7     # corner-hole distance from the outer edges
NOTCH_HOLE_X = 37.5
NOTCH_HOLE_E = 12.2  # distance of notch-side holes from top/bottom edge
SIDE_HOLE_X = 67.6
SIDE_HOLE_Z = 17.1
ODD1 = (-61.5, 76.4)   # holes that repeat with 180 deg symmetry only
ODD2 = (-27.3, 45.3)

SQ = 10.0          # square window size
SQ_R = 2.0         # square window corner radius
SQ_X = 43.8
SQ_Z = 35.3

hx, hz = W / 2.0, H / 2.0

round_holes = []
for sx in (-1, 1):
    for sz in (-1, 1):
        round_holes.append((sx * (hx - E_CORNER), sz * (hz - E_CORNER)))
        round_holes.append((sx * NOTCH_HOLE_X, sz * (hz - NOTCH_HOLE_E)))
        round_holes.append((sx * SIDE_HOLE_X, sz * SIDE_HOLE_Z))
for (px, pz) in (ODD1, ODD2):
    round_holes.append((px, pz))
    round_holes.append((-px, -pz))

square_holes = [(sx * SQ_X, sz * SQ_Z) for sx in (-1, 1) for sz in (-1, 1)]


class NearXZ(cq.Selector):
    """Select edges whose centre lies close to one of the given (x, z) points."""

    def __init__(self, pts, tol=0.6):
        self.pts = pts
        self.tol = tol

    def filter(self, objectList):
        out = []
        for o in objectList:
            c = o.Center()
            for (x, z) in self.pts:
                if abs(c.x - x) < self.tol and abs(c.z - z) < self.tol:
                    out.append(o)
                    break
        return out


# ---------------- base plate ----------------
plate = cq.Workplane("XZ").rect(W, H).extrude(T / 2.0, both=True)

# top & bottom centre notches
for sz in (1, -1):
    cutter = (
        cq.Workplane("XY")
        .box(TN_W, T * 3, TN_D * 2)
        .translate((0, 0, sz * hz))
    )
    plate = plate.cut(cutter)

# side notches
for sx in (1, -1):
    for sz in (1, -1):
        cutter = (
            cq.Workplane("XY")
            .box(SN_D * 2, T * 3, SN_W)
            .translate((sx * hx, 0, sz * SN_Z))
        )
        plate = plate.cut(cutter)

# ---------------- rounding of the outline corners ----------------
corner_pts = [(sx * hx, sz * hz) for sx in (-1, 1) for sz in (-1, 1)]
tn_out_pts = [(sx * TN_W / 2.0, sz * hz) for sx in (-1, 1) for sz in (-1, 1)]
tn_in_pts = [(sx * TN_W / 2.0, sz * (hz - TN_D)) for sx in (-1, 1) for sz in (-1, 1)]
sn_pts = []
for sx in (-1, 1):
    for sz in (-1, 1):
        for dz in (-1, 1):
            z = sz * SN_Z + dz * SN_W / 2.0
            sn_pts.append((sx * hx, z))
            sn_pts.append((sx * (hx - SN_D), z))

plate = plate.edges("|Y").edges(NearXZ(corner_pts)).fillet(R_CORNER)
plate = plate.edges("|Y").edges(NearXZ(tn_out_pts)).fillet(TN_R_OUT)
plate = plate.edges("|Y").edges(NearXZ(tn_in_pts)).fillet(TN_R_IN)
plate = plate.edges("|Y").edges(NearXZ(sn_pts)).fillet(SN_R)

# ---------------- through holes ----------------
# XZ workplane: local x -> global X, local y -> global Z, normal -> -Y
hole_cut = (
    cq.Workplane("XZ", origin=(0, T, 0))
    .pushPoints(round_holes)
    .circle(HOLE_D / 2.0)
    .extrude(T * 2)
)
sq_cut = (
    cq.Workplane("XZ", origin=(0, T, 0))
    .pushPoints(square_holes)
    .sketch()
    .rect(SQ, SQ)
    .vertices()
    .fillet(SQ_R)
    .finalize()
    .extrude(T * 2)
)
result = plate.cut(hole_cut).cut(sq_cut)

# ---------------- bevel on the back of the side tabs ----------------
tab_half = SN_Z - SN_W / 2.0           # tab spans z in [-tab_half, tab_half]
p1 = (hx - BV_X, T / 2.0)              # bevel line on the back face
p2 = (hx, T / 2.0 - BV_Y)              # bevel line on the edge face
dx, dy = p1[0] - p2[0], p1[1] - p2[1]
A = (p1[0] + 0.3 * dx, p1[1] + 0.3 * dy)
B = (p2[0] - 0.3 * dx, p2[1] - 0.3 * dy)
C = (hx + 3.0, T / 2.0 + 3.0)
bevel = (
    cq.Workplane("XY", origin=(0, 0, -tab_half))
    .polyline([A, B, C]).close()
    .extrude(2 * tab_half)
)
bevel = bevel.union(bevel.mirror("YZ"))
result = result.cut(bevel)

VIEW = {"azimuth": 45, "elevation": 26}
